import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
# Frame lies in the XZ plane; front face (with recess + lip) looks to -Y,
# flat back face (with hex nut pockets) at +Y.
W = 120.0          # outer width  (X)
H = 97.8           # outer height (Z)
T = 25.0           # body depth   (Y): front face Y=0, back face Y=T
RC = 5.8           # outer corner radius (in XZ)
RB = 4.0           # fillet on back outer edge

RIM = 3.1          # front rim wall thickness
RIM_R = 3.5        # rim inner corner radius
REC_D = 6.5        # depth of front recess (floor at Y=REC_D)

# raised lip around the window (drafted outer wall)
LIP_H = 3.1        # lip protrusion beyond front face
LIP_W = 88.8       # lip outer width  at its front face
LIP_HH = 67.0      # lip outer height at its front face
LIP_R = 3.5        # lip outer corner radius at its front face
LIP_DRAFT = 15.7   # draft of lip outer wall (deg)
LIP_FRONT_FIL = 0.5  # round on the lip front outer edge

# window / through opening (tapered, widest at the back)
WIN_W = 83.8       # opening width at the lip front face (narrowest)
WIN_H = 61.0
WIN_R = 1.8
BACK_W = 93.0      # opening at back face
BACK_H = 70.6
BACK_R = 2.5
WIN_FIL = 0.6      # round on lip inner front edge
BACK_FIL = 1.5     # fillet on back opening edge

# slots in the recess floor, between rim and lip
SLOT_BOT = 15.4    # Y of top/bottom slot bottoms
SS_BOT = 13.6      # Y of side slot bottoms
SLOT_R = 1.0       # slot corner radius
SLOT_STRIP = 0.4   # floor strip between lip foot and slot
SLOT_IN_FIL = 1.8  # fillet between slot ends and drafted inner wall
TS_X0, TS_X1 = 7.0, 43.3     # top / bottom slots, X range (each side)
TS_ZIN, TS_ZOUT = 34.0, 44.6 # top / bottom slots, Z range (inner side trimmed by lip draft)
SS_Z0, SS_Z1 = 7.3, 32.0     # side slots, Z range (each side)
SS_XIN, SS_XOUT = 44.0, 56.9 # side slots, X range at floor (outer wall flush with rim)
SS_DRAFT = 10.8              # draft of side slot walls

# half-round notches in rim at the side slots
NOTCH_X = 53.2
NOTCH_Z = 24.1
NOTCH_R = 5.45
NOTCH_D = 2.4      # depth from the front face
# snap ramps on the lip side walls (at the notch heights)
SNAP_Y = 3.3       # Y of the ramp step
SNAP_H = 0.6       # ramp height
SNAP_L = 6.3       # ramp length along Z

# corner fixing holes with hex nut pockets on the back
HOLE_OFF = 9.8
HOLE_D = 4.8
HEX_AF = 8.5
HEX_DEPTH = 4.0


def rrect(w, h, r):
    return cq.Sketch().rect(w, h).vertices().fillet(r)


# ---------------- build (local frame: XY = face plane, +Z toward the front) ----------------
# local z = -Y(world); local y = Z(world)
body = (cq.Workplane("XY").workplane(offset=-T)
        .placeSketch(rrect(W, H, RC)).extrude(T))
body = body.faces("<Z").edges().fillet(RB)

# front recess
rec = (cq.Workplane("XY").workplane(offset=-REC_D)
       .placeSketch(rrect(W - 2 * RIM, H - 2 * RIM, RIM_R)).extrude(REC_D + 1))
body = body.cut(rec)

# drafted lip: frustum from the recess floor up to the lip front face
lip_len = REC_D + LIP_H
grow = lip_len * math.tan(math.radians(LIP_DRAFT))
lip = (cq.Workplane("XY").workplane(offset=-REC_D - 0.01)
       .placeSketch(rrect(LIP_W + 2 * grow, LIP_HH + 2 * grow, LIP_R + grow))
       .extrude(lip_len + 0.01, taper=LIP_DRAFT))
lip = lip.faces(">Z").edges().fillet(LIP_FRONT_FIL)
body = body.union(lip)

# small snap ramps on the left/right lip walls (ramp rises toward the back, sharp step)
tdr = math.tan(math.radians(LIP_DRAFT))


def x_wall(z):
    return LIP_W / 2 + (LIP_H - z) * tdr


z1, z2 = LIP_H - 1.0, -SNAP_Y
for sx in (-1, 1):
    for sz in (-1, 1):
        prof = [(x_wall(z1) - 0.3, z1), (x_wall(z2) + SNAP_H, z2), (x_wall(z2) - 0.3, z2)]
        prof = [(sx * px, pz) for px, pz in prof]
        wedge = (cq.Workplane("XZ", origin=(0, sz * NOTCH_Z + SNAP_L / 2, 0))
                 .polyline(prof).close().extrude(SNAP_L))
        body = body.union(wedge)


# slot inner walls run parallel to the drafted lip wall, a narrow floor strip away
g2 = (SLOT_BOT + 1 + LIP_H) * math.tan(math.radians(LIP_DRAFT)) + SLOT_STRIP
lip_keep = (cq.Workplane("XY").workplane(offset=-SLOT_BOT - 1)
            .placeSketch(rrect(LIP_W + 2 * g2, LIP_HH + 2 * g2, LIP_R + g2))
            .extrude(SLOT_BOT + 1 + LIP_H, taper=LIP_DRAFT))


def slot_cutter(cx, cz, w, h, bot, draft=0.0):
    """pocket from the recess floor down to Y=bot; w, h measured at floor level"""
    depth = bot - REC_D
    if draft > 0:
        sh = depth * math.tan(math.radians(draft))
        c = (cq.Workplane("XY").workplane(offset=-bot)
             .center(cx, cz).placeSketch(rrect(w - 2 * sh, h - 2 * sh, SLOT_R))
             .extrude(depth, taper=-draft))
        c = c.union(cq.Workplane("XY").workplane(offset=-REC_D)
                    .center(cx, cz).placeSketch(rrect(w, h, SLOT_R)).extrude(0.5))
    else:
        c = (cq.Workplane("XY").workplane(offset=-bot)
             .center(cx, cz).placeSketch(rrect(w, h, SLOT_R))
             .extrude(depth + 0.5))
    c = c.cut(lip_keep)
    # round the corners where the slot ends meet the drafted inner wall
    side_slot = w < h

    def inner_depth_edge(e):
        # edges running down the slot depth, on the lip side of the slot
        ctr = e.Center()
        if e.BoundingBox().zlen < 0.5 * depth:
            return False
        if side_slot:
            return abs(ctr.x) < abs(cx) - 0.1 * w
        return abs(ctr.y) < abs(cz) - 0.1 * h

    sel = [e for e in c.edges().vals() if inner_depth_edge(e)]
    if sel and SLOT_IN_FIL > 0:
        try:
            c = cq.Workplane("XY").add(c.val().fillet(SLOT_IN_FIL, sel))
        except Exception:
            pass
    return c


for sx in (-1, 1):
    for sz in (-1, 1):
        body = body.cut(slot_cutter(sx * (TS_X0 + TS_X1) / 2, sz * (TS_ZIN + TS_ZOUT) / 2,
                                    TS_X1 - TS_X0, TS_ZOUT - TS_ZIN, SLOT_BOT))
        body = body.cut(slot_cutter(sx * (SS_XIN + SS_XOUT) / 2, sz * (SS_Z0 + SS_Z1) / 2,
                                    SS_XOUT - SS_XIN, SS_Z1 - SS_Z0, SS_BOT, SS_DRAFT))

# shallow half-round notches in the rim beside the side slots
npts = [(sx * NOTCH_X, sz * NOTCH_Z) for sx in (-1, 1) for sz in (-1, 1)]
notch = (cq.Workplane("XY").workplane(offset=-NOTCH_D)
         .pushPoints(npts).circle(NOTCH_R).extrude(NOTCH_D + 0.5))
body = body.cut(notch)

# tapered through opening (narrowest at the lip front face, widest at the back)
open_cut = (cq.Workplane("XY").workplane(offset=-T - 0.01)
            .placeSketch(rrect(BACK_W, BACK_H, BACK_R),
                         rrect(WIN_W, WIN_H, WIN_R).moved(cq.Location(cq.Vector(0, 0, T + LIP_H + 0.02))))
            .loft())
body = body.cut(open_cut)
body = body.faces("<Z").edges(cq.selectors.BoxSelector((-BACK_W / 2 - 1, -BACK_H / 2 - 1, -T - 1),
                                                      (BACK_W / 2 + 1, BACK_H / 2 + 1, -T + 1))).fillet(BACK_FIL)
# rounded inner front edge of the lip
body = body.faces(">Z").edges(cq.selectors.BoxSelector((-WIN_W / 2 - 1, -WIN_H / 2 - 1, LIP_H - 1),
                                                      (WIN_W / 2 + 1, WIN_H / 2 + 1, LIP_H + 1))).fillet(WIN_FIL)

# corner holes + hex pockets on back
hx = W / 2 - HOLE_OFF
hz = H / 2 - HOLE_OFF
pts = [(sx * hx, sz * hz) for sx in (-1, 1) for sz in (-1, 1)]
holes = (cq.Workplane("XY").workplane(offset=-T - 1)
         .pushPoints(pts).circle(HOLE_D / 2).extrude(T + 2))
body = body.cut(holes)
hexes = (cq.Workplane("XY").workplane(offset=-T - 1)
         .pushPoints(pts).polygon(6, HEX_AF / math.cos(math.radians(30)))
         .extrude(HEX_DEPTH + 1))
body = body.cut(hexes)

# orient: local +Z (front) -> world -Y ; local Y -> world Z
result = body.rotate((0, 0, 0), (1, 0, 0), 90)

VIEW = {"azimuth": 45, "elevation": 26}
